import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_IN = 8.8          # ring inner radius
R_OUT = 10.0        # ring outer radius
W_MID = 3.8         # shank width (along Y) at z = 0
W_SLOPE = 0.10      # shank width growth per mm of height
SLOT_TIP_Z = -1.6   # bottom tip of the V slot
SLOT_SLOPE = 0.10   # half-width growth of slot per mm
SHANK_CUT_DEG = 45  # shank ends this many degrees from top dead centre
BAR_Y0, BAR_Y1 = -2.3, -1.3   # strip of the -X shank that runs on under the arch legs
BAR_R_OUT = 9.85
BAR_A0, BAR_A1 = -45.0, -10.0  # its angular extent (deg from top, + towards +X)
POCKET_DEPTH = 0.5  # shallow pocket on the inner face around each V slot
POCKET_Z0, POCKET_HW0 = -2.3, 0.55   # pocket flat bottom height / half width
POCKET_Z1, POCKET_HW1 = 8.0, 1.60    # pocket top height / half width

ARCH_R_OUT = 10.05  # arch strips: same radii as the ring, on shifted axes
END_FILLET = 0.35   # corner rounding of the flat right-leg ends
TAB_Y_SPLIT = -1.4  # below this y the left-leg ends get radial (not vertical) walls
T_W = 1.25          # teardrop band width

H0, H1 = -2.0, 16.0   # vertical extent of the 2D-outline prisms


def cyl_z(cx, cy, r):
    """vertical cylinder (axis // Z) used to build top-view outlines"""
    return (cq.Workplane("XY").workplane(offset=H0)
            .center(cx, cy).circle(r).extrude(H1 - H0))


def lens(cA, rA, cB, rB):
    return cyl_z(cA[0], cA[1], rA).intersect(cyl_z(cB[0], cB[1], rB))


def lens_band(cA, rA, wA, cB, rB, wB):
    return lens(cA, rA, cB, rB).cut(lens(cA, rA - wA, cB, rB - wB))


def cyl_y(xc, zc, r, half=12.0):
    """cylinder with axis parallel to Y through (xc, zc)"""
    return (cq.Workplane("XZ").center(xc, zc).circle(r)
            .extrude(half, both=True))


def shell_y(xc, zc, r_in, r_out):
    return cyl_y(xc, zc, r_out).cut(cyl_y(xc, zc, r_in))


def box(x0, x1, y0, y1, z0=-30, z1=30):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def arc_x(c, r, y, side):
    """x of circle (c, r) at height y; side=-1 left branch, +1 right branch"""
    return c[0] + side * math.sqrt(r * r - (y - c[1]) ** 2)


# ---------------- shank ----------------
tube = (cq.Workplane("XZ").circle(R_OUT).circle(R_IN)
        .extrude(6, both=True))

zb, zt = -11.0, 11.0
wb = W_MID + W_SLOPE * zb
wt = W_MID + W_SLOPE * zt
width_prism = (cq.Workplane("YZ")
               .polyline([(-wb / 2, zb), (wb / 2, zb), (wt / 2, zt), (-wt / 2, zt)])
               .close().extrude(12, both=True))

slot_top = 11.0
sw = SLOT_SLOPE * (slot_top - SLOT_TIP_Z)
slot = (cq.Workplane("YZ")
        .polyline([(-0.06, SLOT_TIP_Z), (0.06, SLOT_TIP_Z), (sw, slot_top), (-sw, slot_top)])
        .close().extrude(12, both=True))

a = math.radians(SHANK_CUT_DEG)
wedge = (cq.Workplane("XZ")
         .polyline([(0, 0), (20 * math.sin(a), 20 * math.cos(a)),
                    (-20 * math.sin(a), 20 * math.cos(a))])
         .close().extrude(12, both=True))

pocket = (cq.Workplane("YZ")
          .polyline([(-POCKET_HW0, POCKET_Z0), (POCKET_HW0, POCKET_Z0),
                     (POCKET_HW1, POCKET_Z1), (-POCKET_HW1, POCKET_Z1)])
          .close().extrude(12, both=True)
          .intersect(cq.Workplane("XZ").circle(R_IN + POCKET_DEPTH).circle(R_IN - 0.5)
                     .extrude(6, both=True)))

shank = tube.intersect(width_prism).cut(slot).cut(pocket).cut(wedge)


def sector_xz(a0, a1, L=20.0):
    """prism along Y covering polar angles a0..a1 (deg from +Z towards +X)"""
    pts = [(0, 0)]
    n = 4
    for i in range(n + 1):
        t = math.radians(a0 + (a1 - a0) * i / n)
        pts.append((L * math.sin(t), L * math.cos(t)))
    return cq.Workplane("XZ").polyline(pts).close().extrude(12, both=True)


bar = (cq.Workplane("XZ").circle(BAR_R_OUT).circle(R_IN).extrude(6, both=True)
       .intersect(box(-20, 20, BAR_Y0, BAR_Y1))
       .intersect(sector_xz(BAR_A0, BAR_A1)))
shank = shank.union(bar)

# ---------------- head ----------------
ring_shell = shell_y(0, 0, R_IN, R_OUT)

# teardrop / leaf loop (lens), lying on the ring surface
T_A, T_RA = (6.13, -1.47), 7.82
T_B, T_RB = (0.35, -0.16), 6.76
teardrop = lens_band(T_A, T_RA, T_W, T_B, T_RB, T_W).intersect(ring_shell)
# its outer (+X) side ends on the same radial plane as the shank, giving that
# flank a radial wall instead of a vertical one
teardrop = teardrop.cut(sector_xz(SHANK_CUT_DEG, 120.0))

# three pointed arches (lens bands trimmed at the legs, rounded leg ends)
arch_defs = [
    # cA (left arc centre), rA, wA, cB (right arc centre), rB, wB,
    # left-leg end y, x limit of that cut, right-leg end angle about cB (deg),
    # axis shift (dx, dz) and dip towards +Y (deg) of the supporting surface
    ((2.70, -0.78), 9.99, 1.30, (-5.00, 1.15), 6.55, 1.35, -2.9, -3.0, -25.0, (0.40, 0.46, 0.0)),
    ((3.35, -1.24), 8.94, 1.10, (-4.02, 1.27), 7.60, 1.50, -2.9, -2.0, -42.0, (0.90, 0.465, 2.5)),
    ((3.17, -1.03), 7.06, 1.15, (-1.44, 1.23), 7.21, 1.45, -2.9, -1.0, -31.0, (1.48, 0.365, 2.7)),
]


def oblique_tab(x_out_l, x_in_l, x_out_s, x_in_s, yl, ys, z_a, k, L=5.0):
    """left-leg end tab: stadium region on the plane z = z_a (widened by k in X
    about its centre) extruded along the ring radius through its centre, so
    its walls are radial and its footprint on the sloping surface stays right"""
    xc = 0.5 * (x_out_l + x_in_l)
    w = x_in_l - x_out_l
    m = lambda x: xc + k * (x - xc)
    body = (cq.Workplane("XY").workplane(offset=z_a)
            .polyline([(m(x_out_l), yl), (m(x_out_s), ys), (m(x_in_s), ys), (m(x_in_l), yl)])
            .close().extrude(0.01).val())
    cap = (cq.Workplane("XY").workplane(offset=z_a).center(xc, yl)
           .ellipse(k * w / 2, w / 2).extrude(0.01).val())
    d = cq.Vector(xc, 0, z_a).normalized()
    out = None
    for shp in (body, cap):
        face = cq.Workplane("XY").add(shp).faces("<Z").val()
        sol = cq.Solid.extrudeLinear(face.translate(d * (-L)), d * (2 * L))
        wp = cq.Workplane("XY").add(sol)
        out = wp if out is None else out.union(wp)
    return out


def wedge_z(c, a0, a1, L=20.0):
    """vertical prism of the angular sector a0..a1 (deg) about point c"""
    pts = [c]
    n = 4
    for i in range(n + 1):
        t = math.radians(a0 + (a1 - a0) * i / n)
        pts.append((c[0] + L * math.cos(t), c[1] + L * math.sin(t)))
    return (cq.Workplane("XY").workplane(offset=H0)
            .polyline(pts).close().extrude(H1 - H0))


head = teardrop
for cA, rA, wA, cB, rB, wB, yl, xs, phi, (dx, dz, tilt) in arch_defs:
    band = lens_band(cA, rA, wA, cB, rB, wB)
    band = band.cut(box(-20, xs, -20, yl)).cut(wedge_z(cB, -95.0, phi))
    # rounded cap on the left-leg end (right-leg end stays a flat radial cut)
    xl = 0.5 * (arc_x(cA, rA, yl, -1) + arc_x(cA, rA - wA, yl, -1))
    band = band.union(cyl_z(xl, yl, wA / 2))
    sh = shell_y(dx, dz, R_IN, ARCH_R_OUT).rotate((dx, 0, dz), (dx + 1, 0, dz), -tilt)
    # left-leg end (tab) re-made with radial side walls
    tab_zone = box(-20, xs, -20, TAB_Y_SPLIT)
    q = math.sqrt(ARCH_R_OUT ** 2 - (xl - dx) ** 2)
    z_a = dz + q - yl * math.tan(math.radians(tilt))
    slope = -(xl - dx) / q                       # dz/dx of the supporting surface
    k = 1.0 + slope * (-xl / z_a)                # footprint compensation
    tab = oblique_tab(arc_x(cA, rA, yl, -1), arc_x(cA, rA - wA, yl, -1),
                      arc_x(cA, rA, TAB_Y_SPLIT, -1), arc_x(cA, rA - wA, TAB_Y_SPLIT, -1),
                      yl, TAB_Y_SPLIT, z_a, k)
    band = band.cut(tab_zone).union(tab)
    arch = band.intersect(sh)
    # round the two vertical corners of the flat right-leg end
    ex = cB[0] + (rB - wB / 2) * math.cos(math.radians(phi))
    ey = cB[1] + (rB - wB / 2) * math.sin(math.radians(phi))
    sel = cq.selectors.BoxSelector((ex - 1.2, ey - 1.2, -20), (ex + 1.2, ey + 1.2, 20))
    try:
        arch = arch.edges("|Z").edges(sel).fillet(END_FILLET)
    except Exception:
        pass
    head = head.union(arch)

result = shank.union(head)
